import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0          # outer width  (X)
L = 134.0         # outer length (Y)
H = 13.4          # body height to outer top ledge
R_OUT = 5.0       # outer vertical corner radius
T_WALL = 3.8      # wall thickness
T_FLOOR = 1.6     # floor thickness
R_IN = 0.5        # cavity vertical corner radius

# tongue (lip) on top of the wall
LIP_H = 1.5       # tongue height above outer ledge
LIP_OUT = 1.2     # tongue outer face inset from outer wall
LIP_IN = 2.85     # tongue inner face inset from outer wall
LIP_R_IN = 0.7    # rounding of the tongue top inner edge
LIP_R_OUT = 0.25  # rounding of the tongue top outer edge

BOSS_D = 4.4      # standoff boss diameter
BOSS_H = 6.7      # boss height above floor
PIN_D = 1.4       # locating pin diameter
PIN_H = 4.5       # pin height above boss
PIN_CH = 0.3      # pin tip chamfer
BOSS_OFF = 6.2    # boss centre offset from outer faces
BOSS_MID_Y = 12.5 # Y position of the mid-side boss (+X side)

# notches in the +Y end wall
LIP_CUT = (-20.6, 6.9)          # X range where tongue is removed
NOTCH1 = (-19.5, -9.8, 4.4)     # x0, x1, depth below ledge
NOTCH2 = (-5.6, 6.2, 5.8)

ZTOP = H + LIP_H


def rrect(inset, r, z0, h):
    """rounded rectangle inset from the outer outline, extruded from z0 by h"""
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .rect(W - 2 * inset, L - 2 * inset)
        .extrude(h)
        .edges("|Z").fillet(r)
    )


# ---------------- shell with tongue ----------------
part = rrect(0, R_OUT, 0, H)
part = part.cut(rrect(T_WALL, R_IN, T_FLOOR, ZTOP))          # cavity
tongue = rrect(LIP_OUT, R_OUT - LIP_OUT, H, LIP_H).cut(
    rrect(LIP_IN, R_OUT - LIP_IN, H, LIP_H)
)
# rounded tongue top: larger round on the cavity side, small on the outside
_ix, _iy = W / 2 - LIP_IN + 0.1, L / 2 - LIP_IN + 0.1
_inner = cq.selectors.BoxSelector((-_ix, -_iy, ZTOP - 0.05), (_ix, _iy, ZTOP + 0.05))
tongue = tongue.edges(_inner).fillet(LIP_R_IN)
tongue = tongue.faces(">Z").edges(cq.selectors.InverseSelector(_inner)).fillet(LIP_R_OUT)
part = part.union(tongue)

# ---------------- bosses with locating pins ----------------
bx = W / 2 - BOSS_OFF
by = L / 2 - BOSS_OFF
boss_pts = [(-bx, by), (bx, by), (bx, BOSS_MID_Y), (-bx, -by), (bx, -by)]

bosses = (
    cq.Workplane("XY", origin=(0, 0, T_FLOOR))
    .pushPoints(boss_pts)
    .circle(BOSS_D / 2)
    .extrude(BOSS_H)
)
pins = (
    cq.Workplane("XY", origin=(0, 0, T_FLOOR + BOSS_H))
    .pushPoints(boss_pts)
    .circle(PIN_D / 2)
    .extrude(PIN_H)
    .faces(">Z").edges().chamfer(PIN_CH)
)
part = part.union(bosses).union(pins)

# ---------------- notches in +Y end wall ----------------
ywall = L / 2 - T_WALL / 2
lip_cut = (
    cq.Workplane("XY", origin=((LIP_CUT[0] + LIP_CUT[1]) / 2, ywall, H))
    .rect(LIP_CUT[1] - LIP_CUT[0], T_WALL + 2)
    .extrude(LIP_H + 1)
)
part = part.cut(lip_cut)

for x0, x1, d in (NOTCH1, NOTCH2):
    n = (
        cq.Workplane("XY", origin=((x0 + x1) / 2, ywall, H - d))
        .rect(x1 - x0, T_WALL + 2)
        .extrude(d + LIP_H + 1)
    )
    part = part.cut(n)

result = part
